import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
H_T = 18.4        # half height of the tube (rear body) outer skin
H_B = 21.0        # half height of the front bracket cap outer skin
T = 1.6           # sheet thickness
R_TUBE = 10.0     # edge round of the tube skin
R_CAP = 6.0       # edge round of the bracket cap along the bulge
R_CAP_LEFT = 4.0  # edge round of the jaws' slanted left edges
CAP_SLOPE = 8.0   # width of the cap's sloping rear rim
JAW = 16.8        # inner face of the fork jaws (|z|)
STRIP = 15.0      # inner face of the raised strips on the jaws (|z|)
FLANGE_Z = (14.9, 12.8)   # lower edge (|z|) of the jaw side flanges, front / rear part
LIP = 8.6         # inner face of the thick rear tongues (|z|)
H_LIP = 18.8      # outer face of the rear tongues (flared rim)
R_LIP = 3.0       # round on the tongue rim
REAR_NUT = (-28.9, 38.1)
TAB_C = (-27.0, 40.0)    # centre of the rear nut boss
R_TAB = 14.0      # radius of the rear nut boss
HEX_AF = 10.6     # hex pocket across flats (flush weld nut)
HEX_DEPTH = 2.0   # hex pocket depth
HOLE_D = 7.0      # bolt hole diameter

PIV = (-5.7, -15.9)                  # front pivot = centre of the bulge arc
R_BULGE = 44.0
ARC_C, ARC_R = (16.9, -23.1), 39.6   # rear boundary of the bracket cap

FORK_L, FORK_R = (-21.8, -14.5), (40.0, -16.9)   # side walls end on this line
OPEN_L, OPEN_R = (-37.8, 23.0), (-4.3, 50.2)     # rear opening line
TOOTH_Y = -39.5                                  # thin tooth in front of this


def arc_pt(ang_deg, r=R_BULGE, c=PIV):
    a = math.radians(ang_deg)
    return (c[0] + r * math.cos(a), c[1] + r * math.sin(a))


def outline_wp(z0):
    """plan outline of the part (top view), as a closed wire on plane z0
    (lines and circular arcs only, so offsets and STEP export stay exact)"""
    a0, a1 = -51.5, 48.0
    wp = (cq.Workplane("XY").workplane(offset=z0)
          .moveTo(-37.4, 42.0)
          .lineTo(-38.4, 26.5)
          .threePointArc((-34.6, 8.2), (-28.5, -9.5))
          .lineTo(-21.8, -14.5).lineTo(-17.9, -21.1).lineTo(-10.8, -28.2)
          .lineTo(1.9, -29.3).lineTo(1.5, -39.5)
          .lineTo(3.0, -42.0).lineTo(8.7, -45.3)
          .lineTo(*arc_pt(a0))
          .threePointArc(arc_pt((a0 + a1) / 2), arc_pt(a1))
          .lineTo(15.1, 28.8).lineTo(2.4, 43.1).lineTo(-4.5, 50.0)
          .lineTo(-14.0, 48.3)
          .threePointArc((-30.4, 47.4), (-37.4, 42.0))
          .close())
    return wp


def prism(pts, z0, z1):
    return (cq.Workplane("XY").workplane(offset=z0)
            .polyline(pts).close().extrude(z1 - z0))


def half_plane(p, q, z0, z1, big=200.0):
    """prism on the right-hand side of the directed line p->q"""
    dx, dy = q[0] - p[0], q[1] - p[1]
    L = math.hypot(dx, dy)
    ux, uy = dx / L, dy / L
    nx, ny = uy, -ux
    a = (p[0] - ux * big, p[1] - uy * big)
    b = (q[0] + ux * big, q[1] + uy * big)
    c = (b[0] + nx * big, b[1] + ny * big)
    d = (a[0] + nx * big, a[1] + ny * big)
    return prism([a, b, c, d], z0, z1)


def on_open_line(e):
    m = e.positionAt(0.5)
    dx, dy = OPEN_R[0] - OPEN_L[0], OPEN_R[1] - OPEN_L[1]
    return abs((m.x - OPEN_L[0]) * dy - (m.y - OPEN_L[1]) * dx) / math.hypot(dx, dy) < 0.3


def is_front_edge(e):
    """sharp sheet edges of the jaws (left diagonal, front edge, step, tooth)"""
    m = e.positionAt(0.5)
    return m.y < -9.0 and math.hypot(m.x - PIV[0], m.y - PIV[1]) < R_BULGE - 0.6


def on_left_jaw_edge(e):
    """the slanted left edges of the jaws (rounded like the rest of the skin)"""
    m = e.positionAt(0.5)
    return m.x < -9.0 and -30.0 < m.y < -8.0


def on_bulge(e):
    m = e.positionAt(0.5)
    return abs(math.hypot(m.x - PIV[0], m.y - PIV[1]) - R_BULGE) < 0.5


def round_edges(wp, radius, select):
    s = wp.val()
    edges = [e for e in s.Edges()
             if abs(e.positionAt(0.5).z) > 1.0 and select(e)
             and not (e.geomType() == "LINE"
                      and abs(e.tangentAt(0.5).z) > 0.99)]
    return cq.Workplane("XY").add(s.fillet(radius, edges))


# ---------------- outer skins ----------------
tube = round_edges(outline_wp(-H_T).extrude(2 * H_T), R_TUBE,
                   lambda e: not is_front_edge(e))

# bracket cap: flat top over the fork, falling off towards the tube on a shallow cone
r_top = ARC_R - CAP_SLOPE
r_mid = r_top + H_B * CAP_SLOPE / (H_B - H_T + 0.2)
cone = (cq.Workplane("XZ")
        .polyline([(0, -H_B), (r_top, -H_B), (r_mid, 0), (r_top, H_B), (0, H_B)]).close()
        .revolve(360, (0, 0, 0), (0, 1, 0)).translate((ARC_C[0], ARC_C[1], 0)))
cap = (outline_wp(-H_B).extrude(2 * H_B)
       .intersect(cq.Workplane("XY").workplane(offset=-H_B).center(*ARC_C)
                  .circle(ARC_R).extrude(2 * H_B))
       .intersect(cone))
cap = round_edges(cap, R_CAP, lambda e: abs(e.positionAt(0.5).z) > H_T and on_bulge(e))
cap = round_edges(cap, R_CAP_LEFT, lambda e: abs(e.positionAt(0.5).z) > H_T
                  and on_left_jaw_edge(e))
body = tube.union(cap)

# round-over of the short straight wall piece in front of the left arc (same radius as
# the tube rounds; built as a swept quarter-round cutter, top and bottom)
def edge_round_cutter(p, q, radius, z_top):
    L = math.dist(p, q)
    ux, uy = (q[0] - p[0]) / L, (q[1] - p[1]) / L
    ang = math.degrees(math.atan2(-ux, uy))            # local +X -> outward normal
    blk = cq.Workplane("XY").box(radius + 1.0, L, radius + 1.0, centered=False)
    blk = blk.translate((-radius, 0, z_top - radius))
    cyl = (cq.Workplane("XZ").center(-radius, z_top - radius).circle(radius)
           .extrude(-L))
    return (blk.cut(cyl).rotate((0, 0, 0), (0, 0, 1), ang)
            .translate((p[0], p[1], 0)))


for zs in (1, -1):
    cutter = edge_round_cutter((-28.5, -9.5), (-21.8, -14.5), R_TUBE, H_T)
    body = body.cut(cutter if zs > 0 else cutter.mirror("XY"))

# ---------------- hollow tube (between fork line and rear opening) ----------------
inner = outline_wp(-(H_T - T)).offset2D(-T).extrude(2 * (H_T - T))
inner = round_edges(inner, R_TUBE - T, lambda e: not is_front_edge(e))
inner_full = inner
inner = (inner.cut(half_plane(FORK_L, FORK_R, -H_B, H_B))      # keep behind fork line
              .cut(half_plane(OPEN_R, OPEN_L, -H_B, H_B)))     # keep in front of opening
body = body.cut(inner)

# ---------------- fork slot: side walls removed, thick jaws remain ----------------
body = body.cut(half_plane(FORK_L, FORK_R, -JAW, JAW))

# thin teeth (one sheet thick) at the very front of both jaws
TOOTH_PTS = [(1.5, TOOTH_Y), (60.0, TOOTH_Y), (60.0, -80.0), (1.5, -80.0)]
body = body.cut(prism(TOOTH_PTS, -(H_B - T), H_B - T))

# bend relief at the inner corner of the jaw step
body = body.cut(cq.Workplane("XY").center(1.0, -31.0).circle(2.0)
                .extrude(2 * (H_B - T)).translate((0, 0, -(H_B - T))))

# raised strips (tube walls running into the fork) on the left part of each jaw
def strip_wp(z0):
    return (cq.Workplane("XY").workplane(offset=z0)
            .moveTo(-29.5, -8.0).lineTo(-21.8, -14.5).lineTo(-17.9, -21.1)
            .lineTo(-10.8, -28.2).lineTo(-2.6, -28.9).lineTo(5.0, -8.5)
            .threePointArc((-1.5, -3.0), (-9.0, -4.5)).close())


for z0, z1 in ((STRIP, JAW + 0.3), (-JAW - 0.3, -STRIP)):
    body = body.union(strip_wp(z0).extrude(z1 - z0).intersect(inner_full))

# short down-turned flanges left of the side wall along the bulge of each jaw
ring = (outline_wp(-H_B).extrude(2 * H_B)
        .cut(outline_wp(-H_B).offset2D(-T).extrude(2 * H_B)))
for y0, y1, zf in ((TOOTH_Y, -27.0, FLANGE_Z[0]), (-27.0, -16.0, FLANGE_Z[1])):
    for sgn in (1, -1):
        z0, z1 = (zf, JAW + 0.3) if sgn > 0 else (-JAW - 0.3, -zf)
        body = body.union(ring.intersect(prism([(12.0, y0), (60.0, y0), (60.0, y1), (12.0, y1)],
                                               z0, z1)))

# ---------------- rear opening (side walls end, thick tongues remain) ----------------
body = body.cut(half_plane(OPEN_R, OPEN_L, -LIP, LIP))
# the rear weld nuts sit in rounded bosses that stand slightly proud of the rim
for sgn in (1, -1):
    z0, z1 = (LIP, H_LIP) if sgn > 0 else (-H_LIP, -LIP)
    tg = (cq.Workplane("XY").workplane(offset=z0).center(*TAB_C)
          .circle(R_TAB).extrude(z1 - z0)
          .intersect(outline_wp(z0).extrude(z1 - z0)))
    ts = tg.val()
    rim = [e for e in ts.Edges() if abs(abs(e.positionAt(0.5).z) - H_LIP) < 0.01]
    body = body.union(cq.Workplane("XY").add(ts.fillet(R_LIP, rim)))

# ---------------- L-shaped stop tabs at the back of the fork (+X side) ----------------
# a front plate facing the slot (bent back at its inner end) and a flange with a hole
inside = outline_wp(-H_T).offset2D(-T * 0.5).extrude(2 * H_T)
TAB_Y = -16.9                      # front face of the tabs
TAB_X0, TAB_X1 = 27.5, 40.0        # flat front plate
TAB_Z0 = 2.6                       # inner edge (|z|) of each tab
tab_plate = [(TAB_X0, TAB_Y), (TAB_X1, TAB_Y), (TAB_X1, TAB_Y + T), (TAB_X0 + 0.7, TAB_Y + T),
             (TAB_X0 - 4.3, TAB_Y + 5.0 + T * 0.7), (TAB_X0 - 5.4, TAB_Y + 4.0)]
tab_flange = [(TAB_X0 - 5.0, TAB_Y + 4.5), (TAB_X0, TAB_Y), (TAB_X1, TAB_Y),
              (TAB_X1, -2.0), (TAB_X0 - 5.0, -2.0)]
for sgn in (1, -1):
    z0, z1 = (TAB_Z0, JAW + 0.5) if sgn > 0 else (-JAW - 0.5, -TAB_Z0)
    f0, f1 = (TAB_Z0, TAB_Z0 + T) if sgn > 0 else (-TAB_Z0 - T, -TAB_Z0)
    tab = prism(tab_plate, z0, z1).union(prism(tab_flange, f0, f1)).intersect(inside)
    body = body.union(tab)
# web joining the two flanges at the back (C-channel)
body = body.union(prism([(TAB_X0 - 9.0, -2.0 - T), (TAB_X1, -2.0 - T), (TAB_X1, -2.0),
                         (TAB_X0 - 9.0, -2.0)], -TAB_Z0 - T, TAB_Z0 + T).intersect(inside))
body = body.cut(cq.Workplane("XY").center(30.5, -9.0).circle(2.2)
                .extrude(2 * JAW).translate((0, 0, -JAW)))

# ---------------- flush weld nuts: hex pockets + bolt holes ----------------
hex_d = HEX_AF / math.cos(math.pi / 6)
NUTS = [(REAR_NUT, H_LIP), (PIV, H_B), ((13.1, -15.0), H_B)]
for (x, y), ztop in NUTS:
    for sgn in (1, -1):
        pocket = (cq.Workplane("XY").polygon(6, hex_d).extrude(HEX_DEPTH + 5.0)
                  .translate((x, y, ztop - HEX_DEPTH)))
        if sgn < 0:
            pocket = pocket.mirror("XY")
        body = body.cut(pocket)
    body = body.cut(cq.Workplane("XY").center(x, y).circle(HOLE_D / 2)
                    .extrude(4 * H_B).translate((0, 0, -2 * H_B)))

result = body
